import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 30.0        # clamp ring outer radius
R_IN = 21.8         # clamp ring bore radius
H = 20.5            # ring height
EAR_HALF = 12.75    # half width (Y) of the clamp ears
SLOT_W = 2.5        # clamp slot width
EAR_END_X = 36.3    # end of the free (+Y) ear
GAP_W = 1.8         # gap between free ear and manifold
SCREW_X = 28.6      # clamp screw axis x
SCREW_D = 6.5       # clamp screw hole diameter
CBORE_R = 6.4       # counterbore radius (-Y side)
CBORE_FLOOR = 7.0   # |y| of counterbore floor
HEX_AF = 11.8       # nut trap across flats (+Y side)
HEX_FLOOR = 9.0     # |y| of nut trap floor

WEB_X0 = 21.3       # web start on ring top
WEB_ANG = 28.5      # web top slope (deg)

HUB_X = 38.4        # manifold hub centre x
SQ = 20.5           # port square size
CYL_D = 24.0        # corner trimming cylinder diameter
SPH_R = 30.7        # end sphere radius (centred on hub)
BORE_D = 13.6       # port bore diameter
BORE_DEPTH = 16.5   # port bore depth
ARM_AZ = 46.0       # azimuth of the inclined ports
ARM_EL = 50.0       # elevation of the inclined ports
ARM_ROLL = -22.0    # roll of the inclined port square about its axis

ZC = H / 2.0
HUB = (HUB_X, 0, ZC)

# ---------------- clamp ring + ears ----------------
ring = cq.Workplane("XY").circle(R_OUT).circle(R_IN).extrude(H)

ears = (cq.Workplane("XY")
        .center((R_IN + HUB_X) / 2.0, 0)
        .rect(HUB_X - R_IN, 2 * EAR_HALF)
        .extrude(H))
body = ring.union(ears)

# sloped web on the fixed (-Y) ear, rising toward the manifold
WEB_X1 = HUB_X + 4.0   # web runs on until it is buried in the inclined port
web_top = H + (WEB_X1 - WEB_X0) * math.tan(math.radians(WEB_ANG))
web = (cq.Workplane("XZ", origin=(0, -SLOT_W / 2.0, 0))
       .polyline([(WEB_X0, H), (WEB_X1, web_top), (WEB_X1, H)]).close()
       .extrude(EAR_HALF - SLOT_W / 2.0))
body = body.union(web)
# keep the clamp bore clean where the web starts on the ring top
body = body.cut(cq.Workplane("XY").circle(R_IN).extrude(H + 40).translate((0, 0, -1)))


# ---------------- manifold ports ----------------
def port_prism(length):
    box = cq.Workplane("YZ").rect(SQ, SQ).extrude(length)
    cyl = cq.Workplane("YZ").circle(CYL_D / 2.0).extrude(length)
    return box.intersect(cyl)


def orient(wp, az, el, roll):
    return (wp.rotate((0, 0, 0), (1, 0, 0), roll)
            .rotate((0, 0, 0), (0, 1, 0), -el)
            .rotate((0, 0, 0), (0, 0, 1), az)
            .translate(HUB))


L = SPH_R + 5
p_x = port_prism(L).translate(HUB)
p_a = orient(port_prism(L), ARM_AZ, ARM_EL, ARM_ROLL)
p_b = orient(port_prism(L), -ARM_AZ, ARM_EL, -ARM_ROLL)
ports = p_x.union(p_a).union(p_b)
sphere = cq.Workplane("XY").sphere(SPH_R).translate(HUB)
ports = ports.intersect(sphere)

body = body.union(ports)

# ---------------- cuts ----------------
# clamp slot (L-shaped: along the ears, then across behind the free ear)
slot = (cq.Workplane("XY")
        .center((15.0 + EAR_END_X + GAP_W) / 2.0, 0)
        .rect(EAR_END_X + GAP_W - 15.0, SLOT_W)
        .extrude(H + 40).translate((0, 0, -1)))
gap = (cq.Workplane("XY")
       .center(EAR_END_X + GAP_W / 2.0, SLOT_W / 2.0 + 15.0)
       .rect(GAP_W, 30.0)
       .extrude(H + 40).translate((0, 0, -1)))
body = body.cut(slot).cut(gap)

# clamp screw hole, counterbore (-Y) and hex nut trap (+Y)
screw_hole = (cq.Workplane("XZ", origin=(0, 40, 0)).center(SCREW_X, ZC)
              .circle(SCREW_D / 2.0).extrude(80))
cbore = (cq.Workplane("XZ", origin=(0, -CBORE_FLOOR, 0)).center(SCREW_X, ZC)
         .circle(CBORE_R).extrude(30))
nut = (cq.Workplane("XZ", origin=(0, HEX_FLOOR, 0)).center(SCREW_X, ZC)
       .polygon(6, HEX_AF / math.cos(math.radians(30)))
       .extrude(-30))
nut = nut.rotate((SCREW_X, 0, ZC), (SCREW_X, 1, ZC), 30)
body = body.cut(screw_hole).cut(cbore).cut(nut)


# viewing direction used only to park the bore seam edges on the hidden side
_CAM = (math.sin(math.radians(45)) * math.cos(math.radians(26)),
        -math.cos(math.radians(45)) * math.cos(math.radians(26)),
        math.sin(math.radians(26)))


def seam_roll(az, el):
    a, e = math.radians(az), math.radians(el)
    h = (-math.sin(a), math.cos(a), 0.0)
    v = (-math.sin(e) * math.cos(a), -math.sin(e) * math.sin(a), math.cos(e))
    hc = sum(p * q for p, q in zip(h, _CAM))
    vc = sum(p * q for p, q in zip(v, _CAM))
    return math.degrees(math.atan2(vc, hc))


def bore(az, el):
    b = (cq.Workplane("YZ").workplane(offset=SPH_R - BORE_DEPTH)
         .circle(BORE_D / 2.0).extrude(BORE_DEPTH + 5))
    return orient(b, az, el, seam_roll(az, el))


body = body.cut(bore(0, 0)).cut(bore(ARM_AZ, ARM_EL)).cut(bore(-ARM_AZ, ARM_EL))

result = body
